import cadquery as cq

# Driving dimensions (mm)
BALL_DIAMETER = 20.0
BALL_PITCH = 25.0      # centre-to-centre spacing along X
BALL_COUNT = 3

r = BALL_DIAMETER / 2.0
x0 = -(BALL_COUNT - 1) * BALL_PITCH / 2.0


def ball(xc):
    # Plain sphere; orient its (purely cosmetic) seam meridian toward the back
    # so it stays out of sight from the default viewing direction.
    s = cq.Solid.makeSphere(r, angleDegrees1=-90, angleDegrees2=90, angleDegrees3=360)
    s = s.rotate((0, 0, 0), (0, 1, 0), 90)    # pole Z -> X, seam +X -> -Z
    s = s.rotate((0, 0, 0), (1, 0, 0), 90)    # seam -Z -> +Y
    s = s.rotate((0, 0, 0), (0, 0, 1), 45)    # pole -> (1,1,0), seam -> (-1,1,0)
    return s.translate(cq.Vector(xc, 0, 0))


balls = [ball(x0 + i * BALL_PITCH) for i in range(BALL_COUNT)]

result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(balls)])

VIEW = {"azimuth": 45, "elevation": 26}
